import math
import itertools
import cadquery as cq
from OCP.BRepBuilderAPI import BRepBuilderAPI_NurbsConvert

# =====================================================================
#  D12 (dodecahedron) enclosure: rounded edges, raised face numbers,
#  hollow shell open at the (sliced) bottom, cable notch in face "5",
#  internal partition, two screw bosses and two rear wall grooves.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
EDGE = 25.0            # dodecahedron edge length
FILLET = 2.5           # outer edge rounding radius
BOTTOM_TRUNC = 3.4     # amount sliced off the bottom face
WALL = 3.7             # shell wall thickness
TEXT_SIZE = 9.0        # number font size
TEXT_RAISE = 0.3       # embossed number height
TEXT_THIN = 0.2        # stroke thinning of the font outline (per side)

NOTCH_W = 18.0         # width of the notch in face "5"
NOTCH_H = 6.5          # height of the notch at the outer face (vertical, from bottom)
NOTCH_H_IN = 5.0       # height of the inner (through) part of the notch
NOTCH_STEP_D = 3.6     # depth of the taller outer part of the notch
NOTCH_FLARE = 1.2      # rounding where the notch walls meet the bottom face
NOTCH_EDGE_R = 1.0     # rounding of the notch outer vertical edges

BOSS_R = 2.8           # screw boss radius
HOLE_R = 0.8           # screw pilot hole radius
BOSS_H = 7.8           # screw boss height
BOSS_POS_R = 14.3      # radial position of the screw bosses (rear corners)

GROOVE_R = 1.8         # rear wall groove radius
GROOVE_H = 4.0         # rear wall groove height
GROOVE_POS_R = 15.3    # radial position of the groove axes

PART_F = -6.5          # partition wall rear face position (towards the rear)
PART_T = 1.5           # partition wall thickness
PART_GAP = 4.4         # free gap under the partition (above the bottom face)

PHI = (1 + 5 ** 0.5) / 2
INRADIUS = EDGE / 2 * PHI ** 2 / math.sqrt(3 - PHI)
ELEV = math.atan(0.5)  # elevation of ring-face normals (26.565 deg)
Z_BOT = -INRADIUS + BOTTOM_TRUNC


def normal(az_deg, up):
    """unit face normal; az measured from -Y (front) towards +X"""
    az = math.radians(az_deg)
    s = 1 if up else -1
    return cq.Vector(math.sin(az) * math.cos(ELEV),
                     -math.cos(az) * math.cos(ELEV),
                     s * math.sin(ELEV))


def polar(r, az_deg):
    az = math.radians(az_deg)
    return (r * math.sin(az), -r * math.cos(az))


# face list: (normal, number label)
FACES = [(cq.Vector(0, 0, 1), "12"), (cq.Vector(0, 0, -1), "1")]
UPPER = {0: "10", 72: "11", 144: "7", 216: "8", 288: "9."}
LOWER = {36: "5", 108: "6.", 180: "2", 252: "3", 324: "4"}
for _az, _t in UPPER.items():
    FACES.append((normal(_az, True), _t))
for _az, _t in LOWER.items():
    FACES.append((normal(_az, False), _t))


def solve3v(n1, n2, n3, d1, d2, d3):
    a = [[n.x, n.y, n.z] for n in (n1, n2, n3)]
    rhs = [d1, d2, d3]

    def det3(m):
        return (m[0][0] * (m[1][1] * m[2][2] - m[1][2] * m[2][1])
                - m[0][1] * (m[1][0] * m[2][2] - m[1][2] * m[2][0])
                + m[0][2] * (m[1][0] * m[2][1] - m[1][1] * m[2][0]))
    det = det3(a)
    if abs(det) < 1e-9:
        return None
    out = []
    for col in range(3):
        m = [row[:] for row in a]
        for r in range(3):
            m[r][col] = rhs[r]
        out.append(det3(m) / det)
    return cq.Vector(*out)


def dodecahedron(d, d_bottom=None):
    """planar-faced dodecahedron (face on top) with inradius d;
    the bottom face plane may be moved with d_bottom"""
    ns = [f[0] for f in FACES]
    ds = [d] * 12
    if d_bottom is not None:
        ds[1] = d_bottom
    verts = []
    for i, j, k in itertools.combinations(range(12), 3):
        p = solve3v(ns[i], ns[j], ns[k], ds[i], ds[j], ds[k])
        if p is None:
            continue
        if all(n.dot(p) <= dd + 1e-6 for n, dd in zip(ns, ds)):
            if not any((p - q).Length < 1e-6 for q in verts):
                verts.append(p)
    faces = []
    for n, dd in zip(ns, ds):
        fv = [v for v in verts if abs(n.dot(v) - dd) < 1e-6]
        c = cq.Vector(0, 0, 0)
        for v in fv:
            c = c + v
        c = c * (1.0 / len(fv))
        u = (fv[0] - c).normalized()
        w = n.cross(u)
        fv.sort(key=lambda v: math.atan2((v - c).dot(w), (v - c).dot(u)))
        wire = cq.Wire.makePolygon(fv + [fv[0]])
        faces.append(cq.Face.makeFromWires(wire))
    return cq.Solid.makeSolid(cq.Shell.makeShell(faces))


def lower_apothem(d, z):
    """horizontal apothem of the lower-ring cross-section at height z"""
    return (d + math.sin(ELEV) * z) / math.cos(ELEV)


# local frame on the bottom: F points out through face "5" (compass az 36),
# S runs along that face's bottom edge.
AZ5 = math.radians(36)
FDIR = (math.sin(AZ5), -math.cos(AZ5))
SDIR = (math.cos(AZ5), math.sin(AZ5))


def fs(f, s):
    return (f * FDIR[0] + s * SDIR[0], f * FDIR[1] + s * SDIR[1])


# ---------------- outer body: rounded dodecahedron, bottom sliced ----------------
body = cq.Workplane("XY").add(dodecahedron(INRADIUS))
body = body.edges().fillet(FILLET)
BIG = 200.0
keep = (cq.Workplane("XY").box(BIG, BIG, BIG, centered=(True, True, False))
        .translate((0, 0, Z_BOT)))
body = body.intersect(keep)

# ---------------- hollow interior, open through the bottom ----------------
cavity = cq.Workplane("XY").add(dodecahedron(INRADIUS - WALL, -Z_BOT + 2.0))
body = body.cut(cavity)

inner_keep = cq.Workplane("XY").add(dodecahedron(INRADIUS - 0.6))

# ---------------- internal partition behind the notch ----------------
pw = [fs(PART_F + PART_T, -40), fs(PART_F + PART_T, 40), fs(PART_F, 40), fs(PART_F, -40)]
partition = (cq.Workplane("XY").polyline(pw).close().extrude(60.0)
             .translate((0, 0, Z_BOT + PART_GAP)))
partition = partition.intersect(inner_keep)
body = body.union(partition)

# ---------------- screw bosses at the two rear corners ----------------
bosses = None
for az_d in (144, 288):
    cx, cy = polar(BOSS_POS_R, az_d)
    ang = math.degrees(math.atan2(cy, cx))
    web = 5.0   # web from the boss out to the corner of the shell
    b = (cq.Workplane("XY")
         .center(*polar(BOSS_POS_R + web / 2, az_d))
         .transformed(rotate=(0, 0, ang))
         .slot2D(web + 2 * BOSS_R, 2 * BOSS_R, 0).extrude(BOSS_H)
         .translate((0, 0, Z_BOT)))
    bosses = b if bosses is None else bosses.union(b)
bosses = bosses.intersect(inner_keep)
body = body.union(bosses)
for az_d in (144, 288):
    cx, cy = polar(BOSS_POS_R, az_d)
    h = (cq.Workplane("XY").center(cx, cy).circle(HOLE_R).extrude(BOSS_H - 1.5)
         .translate((0, 0, Z_BOT - 0.01)))
    body = body.cut(h)

# ---------------- rear wall grooves ----------------
for az_d in (180, 252):
    cx, cy = polar(GROOVE_POS_R, az_d)
    g = (cq.Workplane("XY").center(cx, cy).circle(GROOVE_R).extrude(GROOVE_H + 0.01)
         .translate((0, 0, Z_BOT - 0.01)))
    body = body.cut(g)

# ---------------- notch through face "5" at the bottom ----------------
# inner (through) part with flared bottom corners, plus a taller outer recess
ap_out = lower_apothem(INRADIUS, Z_BOT)
hw, fr = NOTCH_W / 2, NOTCH_FLARE
c45 = 1 - 0.70710678
prof = (cq.Workplane("XZ")
        .moveTo(-hw - fr, -0.5)
        .lineTo(-hw - fr, 0.0)
        .threePointArc((-hw - fr * c45, fr * c45), (-hw, fr))
        .lineTo(-hw, NOTCH_H_IN)
        .lineTo(hw, NOTCH_H_IN)
        .lineTo(hw, fr)
        .threePointArc((hw + fr * c45, fr * c45), (hw + fr, 0.0))
        .lineTo(hw + fr, -0.5)
        .close())
notch = (prof.extrude(-(2 * WALL + 10))          # XZ normal is -Y; extrude towards +Y
         .translate((0, -ap_out - 5, Z_BOT)))
f_step = lower_apothem(INRADIUS, Z_BOT + NOTCH_H) - NOTCH_STEP_D
recess = (cq.Workplane("XY").box(2 * hw, 20.0, NOTCH_H + 0.5, centered=(True, False, False))
          .translate((0, -f_step - 20.0, Z_BOT - 0.5)))
notch = notch.union(recess).rotate((0, 0, 0), (0, 0, 1), 36)
body = body.cut(notch)

# round the two outer vertical edges of the notch (where its walls meet face "5")
N5 = normal(36, False)


def _notch_edge(e):
    c = e.Center()
    s_loc = c.x * SDIR[0] + c.y * SDIR[1]
    on_face = abs(N5.dot(c) - INRADIUS) < 0.05
    return on_face and abs(abs(s_loc) - hw) < 0.05 and c.z > Z_BOT + fr


try:
    sel = [e for e in body.edges().vals() if _notch_edge(e)]
    if sel:
        body = cq.Workplane("XY").add(body.val().fillet(NOTCH_EDGE_R, sel))
except Exception:
    pass

# ---------------- raised numbers on the faces ----------------


def face_plane(n):
    origin = n * INRADIUS
    if abs(n.z) > 0.99:
        xdir = cq.Vector(1, 0, 0) if n.z > 0 else cq.Vector(-1, 0, 0)
    else:
        up = cq.Vector(0, 0, 1)
        upd = (up - n * up.dot(n)).normalized()
        xdir = upd.cross(n)
    return cq.Plane(origin=origin, xDir=xdir, normal=n)


def make_label(label, pl):
    """raised number: font outline thinned by TEXT_THIN, extruded TEXT_RAISE
    above the face plane (starting slightly below it for a clean union)"""
    txt = cq.Compound.makeText(label, TEXT_SIZE, 1.0, font="Arial",
                               halign="center", valign="center")
    sols = []
    for f in txt.Faces():
        if f.geomType() != "PLANE" or abs(f.Center().z) > 1e-6:
            continue
        face = f
        if TEXT_THIN > 0:
            try:
                ow = f.outerWire().offset2D(-TEXT_THIN, "arc")
                iws = []
                for w in f.innerWires():
                    iws += w.offset2D(TEXT_THIN, "arc")
                cand = cq.Face.makeFromWires(ow[0], iws)
                # offset curves do not survive STEP export: convert to NURBS
                cand = cq.Face(BRepBuilderAPI_NurbsConvert(cand.wrapped, True).Shape())
                if cand.isValid() and len(ow) == 1:
                    face = cand
            except Exception:
                face = f
        sols.append(cq.Solid.extrudeLinear(face, cq.Vector(0, 0, TEXT_RAISE + 0.2)))
    comp = cq.Compound.makeCompound(sols).translate(cq.Vector(0, 0, -0.2))
    return comp.moved(cq.Location(pl))


result = body
try:
    labels = []
    for n, label in FACES:
        if label == "1":
            continue   # bottom face is open
        labels.append(make_label(label, face_plane(n)))
    result = body.union(cq.Workplane("XY").add(cq.Compound.makeCompound(labels)))
except Exception:
    result = body

VIEW = {"azimuth": 45, "elevation": 26}
